import cadquery as cq

# Wall-mount holder: C-channel (top flange, vertical wall, bottom flange) with
# vertical cooling/grip ribs on the back, a keyhole in the bottom flange and a
# U-shaped recess in the underside of the top flange.
#
# Axes: X = width, Y = depth (wall back face at Y=0, flanges point to -Y),
#       Z = height (bottom flange underside at Z=0).

# ---------------- driving dimensions (mm) ----------------
W = 40.0            # width along X
H = 83.2            # overall height along Z
T_WALL = 3.1        # vertical wall thickness
T_TOP = 4.25        # top flange thickness
T_BOT = 4.6         # bottom flange thickness
D_TOP = 29.6        # top flange depth, measured from wall back face
D_BOT = 32.1        # bottom flange depth, measured from wall back face
R_TOP_BEND = 0.8    # inner fillet wall / top flange
R_BOT_BEND = 0.9    # inner fillet wall / bottom flange
CH_END = 1.2        # chamfer on the inner edges of the two end faces
CH_FRONT = 1.2      # chamfer on bottom flange front top edge

# back ribs
N_RIBS = 5
RIB_W = 2.62
RIB_P = 8.58        # pitch
RIB_H = 2.6         # protrusion behind wall
RIB_X0 = -W / 2     # first rib starts flush with the -X end

# keyhole in bottom flange
HOLE_R = 12.55
HOLE_Y = -20.7      # hole centre (from wall back face)
SLOT_W = 10.4

# recess under top flange
POCK_R = 9.3        # radius of the recess (below the rim chamfer)
POCK_CH = 1.4       # 45 deg chamfer round the recess rim
POCK_DEPTH = 1.8    # depth into the flange
POCK_FRONT = -29.0  # y of the front-most point of the recess rim
POCK_BELOW = 1.2    # bend-fillet clearing cut reaches this far below the underside
POCK_BACK_R = 1.4   # blend between recess floor and wall face

EPS = 0.01
Z_UNDER = H - T_TOP  # top flange underside


def box_sel(p0, p1):
    return cq.selectors.BoxSelector(p0, p1)


# ---------------- body: top flange + wall (extruded L profile) ----------------
body = (
    cq.Workplane("YZ", origin=(-W / 2, 0, 0))
    .polyline([
        (0, 0), (0, H), (-D_TOP, H), (-D_TOP, Z_UNDER),
        (-T_WALL, Z_UNDER), (-T_WALL, 0)
    ]).close()
    .extrude(W)
)

# small inner bend fillet (wall / top flange)
body = body.edges(box_sel(
    (-W, -T_WALL - EPS, Z_UNDER - EPS), (W, -T_WALL + EPS, Z_UNDER + EPS)
)).fillet(R_TOP_BEND)

# chamfer the inner edges of both end faces
# (top flange underside edge + bend + wall inner edge form one chain)
for xs in (-W / 2, W / 2):
    body = body.edges(box_sel(
        (xs - EPS, -D_TOP + EPS, -1.0), (xs + EPS, -T_WALL + EPS, Z_UNDER + EPS)
    )).chamfer(CH_END)

# ---------------- bottom flange ----------------
bot = (cq.Workplane("XY")
       .box(W, D_BOT, T_BOT, centered=(True, False, False))
       .translate((0, -D_BOT, 0)))
body = body.union(bot)

# inner bend fillet (wall / bottom flange)
body = body.edges(box_sel(
    (-W, -T_WALL - EPS, T_BOT - EPS), (W, -T_WALL + EPS, T_BOT + EPS)
)).fillet(R_BOT_BEND)

# chamfer on the front top edge of the bottom flange
body = body.edges(box_sel(
    (-W, -D_BOT - EPS, T_BOT - EPS), (W, -D_BOT + EPS, T_BOT + EPS)
)).chamfer(CH_FRONT)

# keyhole: round hole + straight slot open to the front
slot_len = abs(-D_BOT - 5.0 - HOLE_Y)
keyhole = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .center(0, HOLE_Y).circle(HOLE_R).extrude(T_BOT + 2.0)
    .union(
        cq.Workplane("XY", origin=(0, 0, -1.0))
        .center(0, HOLE_Y - slot_len / 2).rect(SLOT_W, slot_len).extrude(T_BOT + 2.0)
    )
)
body = body.cut(keyhole)

# ---------------- back ribs (full height) ----------------
for i in range(N_RIBS):
    x0 = RIB_X0 + i * RIB_P
    rib = (cq.Workplane("XY")
           .box(RIB_W, RIB_H + 0.01, H, centered=False)
           .translate((x0, -0.01, 0)))
    body = body.union(rib)

# ---------------- recess under top flange ----------------
# U shape: round end towards the front, straight sides running back to the wall.
pc_y = POCK_FRONT + POCK_R + POCK_CH   # centre of the round end


def u_profile(wp, r):
    return (wp.moveTo(-r, -T_WALL)
            .lineTo(-r, pc_y)
            .threePointArc((0, pc_y - r), (r, pc_y))
            .lineTo(r, -T_WALL)
            .close())


# clear the small wall/flange bend fillet over the width of the recess rim
LIP_EXT = 0.2
clear = (cq.Workplane("XY")
         .box(2 * (POCK_R + POCK_CH + LIP_EXT), 2.0, POCK_BELOW, centered=(True, False, False))
         .translate((0, -T_WALL - 2.0, Z_UNDER - POCK_BELOW)))
body = body.cut(clear)

# main cutter; its back/top edge is rounded so the recess floor blends into
# the wall face
z0 = Z_UNDER - 0.3
tool = u_profile(cq.Workplane("XY", origin=(0, 0, z0)), POCK_R).extrude(0.3 + POCK_DEPTH)
tool = tool.edges(box_sel(
    (-W, -T_WALL - EPS, Z_UNDER + POCK_DEPTH - EPS), (W, -T_WALL + EPS, Z_UNDER + POCK_DEPTH + EPS)
)).fillet(POCK_BACK_R)
body = body.cut(tool)

# 45 deg chamfer round the rim of the recess (lofted lip cutter)
lip_bot = u_profile(cq.Workplane("XY", origin=(0, 0, Z_UNDER - LIP_EXT)),
                    POCK_R + POCK_CH + LIP_EXT).wires().val()
lip_top = u_profile(cq.Workplane("XY", origin=(0, 0, Z_UNDER + POCK_CH)), POCK_R).wires().val()
lip = cq.Workplane("XY").add(cq.Solid.makeLoft([lip_bot, lip_top], True))
body = body.cut(lip)

result = body
